import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 5.0              # plate thickness
POCKET_D = 3.0       # depth of the end pockets (from top face)

HALF_W = 100.0       # half width of wide middle section (X)
HALF_L = 120.0       # half overall length (Y)
SHOULDER_Y = 60.0    # |Y| where wide section ends
SHOULDER_X = 78.8    # |X| of shoulder vertex where taper starts
END_HALF_W = 43.0    # half width of narrow ends at |Y| = HALF_L
OUTLINE_R = 7.0      # vertical edge fillet of outline

WIN_R = 1.5          # corner radius of the window inside the end pocket

HOLE_D = 4.0         # small screw holes
HOLE_D2 = 4.7        # slightly larger holes (right side pair)
SLOT_HOLE_D = 7.0    # holes in the end slots

SLOT_W = 12.6        # width of the U slots at the ends
SLOT_X = 33.7        # |X| of slot centre line
SLOT_END_Y = 99.5    # |Y| of slot round-end centre

CP_HALF_W = 21.7     # central pocket (+Y end) half width
CP_Y0 = 98.4         # central pocket inner edge (and lower hole row)
CP_HOLE_X = 16.6
CP_HOLE_Y1 = 98.4
CP_HOLE_Y2 = 112.0
CP_RECT = (-0.2, 109.0, 24.2, 13.4)   # cx, cy, w, h of the through window

# through rectangular cut-outs: (cx, cy, w, h, r)
RECTS = [
    (0.0, 53.2, 106.4, 53.8, 7.0),        # big upper window
    (-25.1, -13.4, 79.5, 26.8, 3.5),      # middle window
    (0.0, -68.7, 106.4, 33.2, 6.0),       # lower window
    (-85.4, 0.0, 16.0, 107.0, 4.0),       # long side slot
    (77.2, 31.9, 16.2, 26.6, 3.0),        # small right window
    (77.2, -44.1, 34.5, 26.6, 4.2),       # square right window
]

SMALL_HOLES = [
    (-17.5, 86.2), (60.0, 86.2),
    (-17.5, 20.1), (60.0, 20.1),
    (-64.0, 5.3), (10.7, 5.3), (-64.0, -32.0), (10.7, -32.0),
    (-39.3, -46.5), (39.4, -46.5),
    (-39.3, -91.4), (39.4, -91.4),
    (-CP_HOLE_X, CP_HOLE_Y1), (CP_HOLE_X, CP_HOLE_Y1),
    (-CP_HOLE_X, CP_HOLE_Y2), (CP_HOLE_X, CP_HOLE_Y2),
]
MID_HOLES = [(63.7, 0.0), (90.3, 0.0)]
SLOT_HOLES = [(sx * SLOT_X, sy * 110.3) for sx in (-1, 1) for sy in (-1, 1)]

# ---------------- outline ----------------
pts = [
    (-HALF_W, -SHOULDER_Y), (-SHOULDER_X, -SHOULDER_Y), (-END_HALF_W, -HALF_L),
    (END_HALF_W, -HALF_L), (SHOULDER_X, -SHOULDER_Y), (HALF_W, -SHOULDER_Y),
    (HALF_W, SHOULDER_Y), (SHOULDER_X, SHOULDER_Y), (END_HALF_W, HALF_L),
    (-END_HALF_W, HALF_L), (-SHOULDER_X, SHOULDER_Y), (-HALF_W, SHOULDER_Y),
]
plate = cq.Workplane("XY").polyline(pts).close().extrude(T)
plate = plate.edges("|Z").fillet(OUTLINE_R)

# ---------------- through windows ----------------
for (cx, cy, w, h, r) in RECTS:
    cutter = (cq.Workplane("XY").center(cx, cy).rect(w, h).extrude(T * 3)
              .translate((0, 0, -T)).edges("|Z").fillet(r))
    plate = plate.cut(cutter)

cx, cy, w, h = CP_RECT
win = (cq.Workplane("XY").center(cx, cy).rect(w, h).extrude(T * 3)
       .translate((0, 0, -T)).edges("|Z").fillet(WIN_R))
plate = plate.cut(win)

# ---------------- end pockets (from the top face) ----------------
z0 = T - POCKET_D
ext = 10.0
pock = None
for sxs in (-1, 1):
    for sys_ in (-1, 1):
        x = sxs * SLOT_X
        yend = sys_ * SLOT_END_Y
        ylen = HALF_L + ext - SLOT_END_Y
        rect = (cq.Workplane("XY").workplane(offset=z0)
                .center(x, sys_ * (SLOT_END_Y + ylen / 2)).rect(SLOT_W, ylen)
                .extrude(POCKET_D + 1))
        circ = (cq.Workplane("XY").workplane(offset=z0)
                .center(x, yend).circle(SLOT_W / 2).extrude(POCKET_D + 1))
        slot = rect.union(circ)
        pock = slot if pock is None else pock.union(slot)

lobe_r = CP_HALF_W - CP_HOLE_X          # lobes tangent to the pocket side walls
ytop = HALF_L + ext
cp = (cq.Workplane("XY").workplane(offset=z0)
      .moveTo(-CP_HALF_W, ytop)
      .lineTo(-CP_HALF_W, CP_Y0)
      .threePointArc((-CP_HOLE_X, CP_Y0 - lobe_r), (-CP_HOLE_X + lobe_r, CP_Y0))
      .lineTo(CP_HOLE_X - lobe_r, CP_Y0)
      .threePointArc((CP_HOLE_X, CP_Y0 - lobe_r), (CP_HALF_W, CP_Y0))
      .lineTo(CP_HALF_W, ytop)
      .close()
      .extrude(POCKET_D + 1))
pock = pock.union(cp)
plate = plate.cut(pock)

# ---------------- holes ----------------
def drill(body, pts_, d):
    c = (cq.Workplane("XY").pushPoints(pts_).circle(d / 2).extrude(T * 3)
         .translate((0, 0, -T)))
    return body.cut(c)

plate = drill(plate, SMALL_HOLES, HOLE_D)
plate = drill(plate, MID_HOLES, HOLE_D2)
plate = drill(plate, SLOT_HOLES, SLOT_HOLE_D)

result = plate
VIEW = {"azimuth": 45, "elevation": 26}
